import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 360.0          # overall length (X)
W = 150.0          # overall width (Y)
H = 9.3            # overall height (top plateau)
H_WALL = 2.5       # vertical outer edge height
BEV_X = 11.5       # bevel run on the short (X) ends
BEV_Y = 16.5       # bevel run on the long (Y) sides
R_OUT = 4.0        # plan corner radius of outer outline
R_NOSE = 1.5       # round-over between outer wall and bevel
R_SOFT = 0.0       # optional soft blend between bevel and flat top (0 = crisp)
T = 2.0            # skin / wall thickness of the moulding

# opening
OP_X = 148.5       # half length of main opening
OP_Y0 = -49.7      # front edge of opening
OP_Y1 = 30.0       # back edge of main opening
EXT_X = 120.0      # half length of rear extension
EXT_Y1 = 50.0      # back edge of rear extension
R_OPEN = 1.0       # small corner radius of the opening outline
LIP_W = 2.0        # inner lip wall thickness
LIP_H = 3.7        # inner lip depth below top (long sides)
END_WALL_EXT = 7.0 # full-height end walls run this far behind the rear edge

# corner pocket (right-rear)
PK_PLATE = 4.0     # corner plate depth below top (its edge shows in the opening)
PK_REC = 2.5       # depth of the rounded recess
PK_R = 2.0         # recess corner radius
PK_IN_OPEN = 2.5   # recess inset from the opening-side edges
PK_IN_WALL = 0.6   # recess inset from the frame-side edges
PK_BOSS_X = 136.0  # screw boss centre
PK_BOSS_Y = 42.0
PK_BOSS_R = 6.0    # screw boss radius
PK_LOBE_R = 2.5    # small side lobe radius
PK_BOSS_TOP = 0.4  # boss top below the frame top

# hanging snap tabs along the rear inner edge
TAB_T = 1.5
TAB_SET = 0.3      # tabs set back from the opening edge
TAB_DEPTH = 7.1    # bottom of tabs below top
TABS = [(-71.0, -18.0), (23.0, 75.0)]
SHORT_TAB = 9.0    # short tabs at the ends of the rear extension

# underside ribs
RIB_T = 1.0        # gusset thickness
RIB_PITCH = 11.0   # gusset pitch under the long-side bevels
RIB_BOT = 0.6      # bottom height of gussets
LRIB_BOT = 0.6     # bottom height of longitudinal ribs
RIB_Y = 61.5       # longitudinal rib position (|y|)
RIB_X = 167.0      # end rib position (|x|)
PAD_BOT = 1.0      # bottom of the solid corner pads
LRIB_T = 1.6       # longitudinal rib thickness
BOSS_END = (12.0, 26.0, 2.0)   # end-border bosses: size x, size y, bottom height

VIEW = {"azimuth": 45, "elevation": 26}


def beveled_block(hx, hy, z0, zw, zt, bx, by, r):
    """Rounded-corner block from z0 to zt whose top edges are bevelled:
    vertical wall up to zw, then planar bevels of run bx (X ends) / by (Y sides)."""
    blk = (
        cq.Workplane("XY")
        .sketch().rect(2 * hx, 2 * hy).vertices().fillet(r).finalize()
        .extrude(zt - z0)
        .translate((0, 0, z0))
    )
    big = 50.0
    sy = (zt - zw) / by
    sx = (zt - zw) / bx
    py = [
        (hy - by - big, zt + big * sy),
        (hy + big, zw - big * sy),
        (hy + big, zt + big * sy + 10),
        (hy - by - big, zt + big * sy + 10),
    ]
    cut_y = (
        cq.Workplane("YZ")
        .polyline(py).close()
        .extrude(2 * hx + 40)
        .translate((-hx - 20, 0, 0))
    )
    px = [
        (hx - bx - big, zt + big * sx),
        (hx + big, zw - big * sx),
        (hx + big, zt + big * sx + 10),
        (hx - bx - big, zt + big * sx + 10),
    ]
    cut_x = (
        cq.Workplane("XZ")
        .polyline(px).close()
        .extrude(-(2 * hy + 40))
        .translate((0, -hy - 20, 0))
    )
    for c in (cut_y, cut_y.mirror("XZ"), cut_x, cut_x.mirror("YZ")):
        blk = blk.cut(c)
    return blk


def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY")
        .center((x0 + x1) / 2, (y0 + y1) / 2)
        .rect(x1 - x0, y1 - y0)
        .extrude(z1 - z0)
        .translate((0, 0, z0))
    )


def rects(items, z0, z1):
    """Many axis-aligned rectangles (cx, cy, sx, sy) extruded together."""
    sk = cq.Sketch()
    for (cx, cy, sx_, sy_) in items:
        sk = sk.push([(cx, cy)]).rect(sx_, sy_).reset()
    return cq.Workplane("XY").placeSketch(sk.clean()).extrude(z1 - z0).translate((0, 0, z0))


# ---------------- outer body ----------------
body = beveled_block(L / 2, W / 2, 0.0, H_WALL, H, BEV_X, BEV_Y, R_OUT)

# round-over between the outer wall and the bevel
body = body.edges(
    cq.selectors.BoxSelector((-L, -W, H_WALL - 0.01), (L, W, H_WALL + 1.0))
).fillet(R_NOSE)
if R_SOFT > 0:
    body = body.edges(cq.selectors.BoxSelector((-L, -W, H - 0.01), (L, W, H + 0.01))).fillet(R_SOFT)

# ---------------- hollow underside ----------------
sy = (H - H_WALL) / BEV_Y
sx = (H - H_WALL) / BEV_X
ky = T * math.sqrt(1 + sy * sy)
kx = T * math.sqrt(1 + sx * sx)
zw_c = H_WALL + T * sy - ky            # cavity wall height at inner skirt face
by_c = (H - H_WALL - T + ky) / sy - T
bx_c = (H - H_WALL - T + kx) / sx - T
cavity = beveled_block(
    L / 2 - T, W / 2 - T, -1.0, zw_c, H - T, bx_c, by_c, max(R_OUT - T, 0.5)
)
body = body.cut(cavity)

# ---------------- underside ribs (inside the hollow) ----------------
hx_in = L / 2 - T + 0.2
hy_in = W / 2 - T + 0.2
rib_items = []
# transverse gussets under the long-side bevels
n = int((L / 2 - BEV_X - 4.0) // RIB_PITCH)
glen = hy_in - RIB_Y
for i in range(-n, n + 1):
    x = i * RIB_PITCH
    for sgn in (-1, 1):
        rib_items.append((x, sgn * (RIB_Y + glen / 2), RIB_T, glen))
ribs = rects(rib_items, RIB_BOT, H - 0.5)
# longitudinal ribs under the long sides and under the short ends
lr = [(0.0, sgn * RIB_Y, 2 * hx_in, LRIB_T) for sgn in (-1, 1)]
lr += [(sgn * RIB_X, 0.0, LRIB_T, 2 * hy_in) for sgn in (-1, 1)]
ribs = ribs.union(rects(lr, LRIB_BOT, H - 0.5))
# solid corner pads where the long sides meet the short ends
pads = []
for sx_ in (-1, 1):
    for sy_ in (-1, 1):
        cx = sx_ * (OP_X + LIP_W + RIB_X) / 2
        cy = sy_ * (RIB_Y + hy_in) / 2
        pads.append((cx, cy, RIB_X - OP_X - LIP_W, hy_in - RIB_Y))
ribs = ribs.union(rects(pads, PAD_BOT, H - 0.5))
# end borders: a central boss and a full-height inner wall
bxs, bys, bzb = BOSS_END
for sgn in (-1, 1):
    xb0 = sgn * (OP_X + LIP_W + bxs / 2 - 0.2)
    ribs = ribs.union(box(xb0 - bxs / 2, xb0 + bxs / 2, -bys / 2, bys / 2, bzb, H - 0.5))
    # full-height inner wall along the short ends of the opening
    xa, xb = sorted((sgn * OP_X, sgn * (OP_X + LIP_W)))
    ribs = ribs.union(box(xa, xb, OP_Y0, OP_Y1 + END_WALL_EXT, 0.0, H - 0.5))
# keep ribs inside the outer envelope only
env = beveled_block(L / 2 - 0.3, W / 2 - 0.3, -1.0, H_WALL - 0.3, H - 0.3, BEV_X, BEV_Y, R_OUT)
ribs = ribs.intersect(env)
body = body.union(ribs)

# ---------------- opening ----------------
open_pts = [
    (-OP_X, OP_Y0),
    (OP_X, OP_Y0),
    (OP_X, OP_Y1),
    (EXT_X, OP_Y1),
    (EXT_X, EXT_Y1),
    (-EXT_X, EXT_Y1),
    (-EXT_X, OP_Y1),
    (-OP_X, OP_Y1),
]


def opening_prism(z0, z1, grow=0.0):
    sk = cq.Sketch().polygon(open_pts + [open_pts[0]]).vertices().fillet(R_OPEN)
    w = cq.Workplane("XY").placeSketch(sk).extrude(z1 - z0)
    if grow:
        w2 = (
            cq.Workplane("XY")
            .add(w.faces("<Z").wires().vals())
            .toPending()
            .offset2D(grow, "arc")
            .extrude(z1 - z0)
        )
        w = w2
    return w.translate((0, 0, z0))


# inner lip around the opening
lip = opening_prism(H - LIP_H, H - 0.5, LIP_W).cut(opening_prism(H - LIP_H - 1, H + 1))
body = body.union(lip)

# corner pocket (right-rear): solid plate under the corner, cut after the opening
pk_x0, pk_x1 = EXT_X, OP_X
pk_y0, pk_y1 = OP_Y1, EXT_Y1
body = body.union(box(pk_x0, pk_x1 + T, pk_y0, pk_y1 + T, H - PK_PLATE, H - 0.5))

# cut the opening through everything
body = body.cut(opening_prism(-2, H + 2))

# rounded recess in the corner plate with a screw boss (round with a small side lobe)
rec = (
    cq.Workplane("XY")
    .sketch()
    .push([((pk_x0 + PK_IN_OPEN + pk_x1 - PK_IN_WALL) / 2,
            (pk_y0 + PK_IN_OPEN + pk_y1 - PK_IN_WALL) / 2)])
    .rect(pk_x1 - pk_x0 - PK_IN_OPEN - PK_IN_WALL, pk_y1 - pk_y0 - PK_IN_OPEN - PK_IN_WALL)
    .reset()
    .vertices()
    .fillet(PK_R)
    .finalize()
    .extrude(PK_REC + 1)
    .translate((0, 0, H - PK_REC))
)
body = body.cut(rec)
boss_h = PK_REC - PK_BOSS_TOP
boss = (
    cq.Workplane("XY")
    .pushPoints([(PK_BOSS_X, PK_BOSS_Y)])
    .circle(PK_BOSS_R)
    .extrude(boss_h)
    .union(
        cq.Workplane("XY")
        .pushPoints([(PK_BOSS_X - 4.6, PK_BOSS_Y - 4.4)])
        .circle(PK_LOBE_R)
        .extrude(boss_h)
    )
    .translate((0, 0, H - PK_REC))
)
body = body.union(boss)

# ---------------- hanging tabs ----------------
tab_items = []
spans = list(TABS) + [(-EXT_X + R_OPEN, -EXT_X + SHORT_TAB)]
for (xa, xb) in spans:
    # snap tabs hang below the lip along the rear edge of the opening only
    yy = EXT_Y1 + TAB_SET
    tab_items.append(((xa + xb) / 2, yy + TAB_T / 2, xb - xa, TAB_T))
tabs = rects(tab_items, H - TAB_DEPTH, H - LIP_H + 0.5)
body = body.union(tabs)

result = body
